import math
import cadquery as cq

# ------------------------------------------------------------------ dimensions
H = 16.0            # half height of the housing (Z)
# +Y extent of the housing along X (slightly curved taper)
W_SECT = [(0.0, 32.4), (40.0, 34.6), (80.0, 38.0)]
X_WALL0 = 6.3       # -X end of the housing behind the lobes

# ribbed -Y side panel (part of the housing section)
PANEL_Y = 1.4       # flat face of the panel

# concave end arc that trims the +X end (axis Z)
END_CX, END_CY, END_R = 104.3, 12.0, 37.0
END_FILLET = 3.0

# lobes / lips at the -X end
LOBE_C = (10.5, 17.1)
LOBE_R = 10.5
LIP_T = 4.0
LIP_IN = H - LIP_T               # inner face of the lips
LOBE_CH_R = 5.0                  # flat bottom radius of the lobe chamfer cone
LOBE_SKIN = 1.5                  # thickness of the lobe rim under the domed top
LOBE_CH_SLOPE = 2.2              # radial run per unit height of the lobe chamfer cone
LOBE_RND = 1.5                   # rounding of the lobe's top rim
EYE_RING = (4.5, 0.8)            # eyelet ring boss: outer radius, height
POCKET_X1 = 19.0                 # back of the open pocket
LIP_EDGE_Y = 7.0                 # -Y edge of the lips in front of the panel
LIP_NOSE_R = 0.85                # rounding of the lip's lower -Y edge
WALL_T = 2.5                     # +Y wall thickness at the pocket
EYE_D = 4.4
PANEL_X1 = 67.94                 # +X end of the panel at the seam (end arc)
PANEL_END = 4.5                  # run-out length of the panel end rounding

# ribs
RIB_N = 8
RIB_X0 = 26.7
RIB_PITCH = 4.64
RIB_HALF = 8.0
RIB_W = 1.35                     # half width (X)
RIB_H = 1.9                      # height (-Y)

# lugs
LUG_Z0, LUG_Z1 = 10.1, 12.9
LUG_HEAD = (74.0, 100.0, -1.0, 30.0)   # x0, x1, y0, y1
LUG_HEAD_R = 12.5
LUG_BLEND = 5.0                        # neck-to-head blend radius
LUG_NECK = (64.0, 82.0, 7.5, 27.0)
LUG_HOLE = (87.2, 16.9)
LUG_HOLE_D = 4.5
BOSS_D = 10.0
BOSS_H = 1.4
NOTCH_C = (75.0, 27.0)
NOTCH_R = 4.0
POST_C = (74.5, 15.35)
POST_R = 2.95
SLOTS = [(16.4, 23.5, 1.1), (16.4, 18.3, 2.5)]   # (y0, y1, half height)

# bottom dimple
DIMPLE = (41.0, 10.0)
DIMPLE_D = 5.5
DIMPLE_DEPTH = 3.5               # measured from Z = -H

# ------------------------------------------------------------------ section
BASE_W = 37.6
SEAM = (5.4, 12.9)                # (Y, Z) crease between the side panel and the hood
T_SEAM = (3.0 * math.cos(math.radians(28)), 3.0 * math.sin(math.radians(28)))
# control polygon of the side panel (flat between the two corner roundings)
SIDE_POLES = [SEAM, (2.6, 12.35), (PANEL_Y, 10.5), (PANEL_Y, 6.0), (PANEL_Y, 0.0)]

# domed hood (measured from the end view silhouette)
TOP_PTS = [(7.1, 13.7), (8.9, 14.5), (11.5, 15.05), (14.3, 15.5), (17.2, 15.85),
           (20.0, 15.78), (22.7, 15.4), (28.3, 14.05), (32.0, 12.0), (35.0, 9.0),
           (36.8, 5.3), (BASE_W, 0.0)]


def _params(pts):
    d = [0.0]
    for a, b in zip(pts[:-1], pts[1:]):
        d.append(d[-1] + math.hypot(b[0] - a[0], b[1] - a[1]))
    return [v / d[-1] for v in d]


PAR_TOP = _params([SEAM] + TOP_PTS)
PAR_BOT = _params([(y, -z) for (y, z) in reversed([SEAM] + TOP_PTS)])


def _scaled(pts, w, zs=1.0):
    s = (w - 17.0) / (BASE_W - 17.0)
    out = []
    for (y, z) in pts:
        if y > 17.0:
            y = 17.0 + (y - 17.0) * s
        out.append((y, z * zs))
    return out


def _bspline(poles3d, degree=3):
    """clamped uniform B-spline edge through a control polygon"""
    from OCP.TColgp import TColgp_Array1OfPnt
    from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
    from OCP.Geom import Geom_BSplineCurve
    from OCP.gp import gp_Pnt
    from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
    n = len(poles3d)
    arr = TColgp_Array1OfPnt(1, n)
    for i, p in enumerate(poles3d):
        arr.SetValue(i + 1, gp_Pnt(*p))
    nk = n - degree + 1
    knots = TColStd_Array1OfReal(1, nk)
    mults = TColStd_Array1OfInteger(1, nk)
    for i in range(nk):
        knots.SetValue(i + 1, i / (nk - 1))
        mults.SetValue(i + 1, degree + 1 if i in (0, nk - 1) else 1)
    crv = Geom_BSplineCurve(arr, knots, mults, degree)
    return cq.Edge(BRepBuilderAPI_MakeEdge(crv).Edge())


def section_wire(x, w, zs=1.0):
    """housing cross-section at station x (in the plane X = x)"""
    def P(y, z):
        return cq.Vector(x, y, z)

    half = [(y, z * zs) for (y, z) in SIDE_POLES]
    poles = [(x, y, -z) for (y, z) in half] + [(x, y, z) for (y, z) in reversed(half[:-1])]
    side = _bspline(poles)
    top = [(SEAM[0], SEAM[1] * zs)] + _scaled(TOP_PTS, w, zs)
    bot = _scaled([(y, -z) for (y, z) in reversed(TOP_PTS[:-1])], w, zs) + [(SEAM[0], -SEAM[1] * zs)]
    bot = [top[-1]] + bot
    e_top = cq.Edge.makeSpline([P(*p) for p in top],
                               tangents=[cq.Vector(0, *T_SEAM), cq.Vector(0, 0, -3)],
                               parameters=PAR_TOP, scale=False)
    e_bot = cq.Edge.makeSpline([P(*p) for p in bot],
                               tangents=[cq.Vector(0, 0, -3), cq.Vector(0, -T_SEAM[0], T_SEAM[1])],
                               parameters=PAR_BOT, scale=False)
    return cq.Wire.assembleEdges([side, e_top, e_bot])


def section_prism(x0, x1, w, zs=1.0):
    wire = section_wire(x0, w, zs)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(wire, [], cq.Vector(x1 - x0, 0, 0)))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False) \
        .translate((x0, y0, z0))


def zcyl(cx, cy, r, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).center(cx, cy) \
        .circle(r).extrude(z1 - z0)


# ------------------------------------------------------------------ housing
body = cq.Workplane("XY").add(
    cq.Solid.makeLoft([section_wire(x, w) for (x, w) in W_SECT], False))

# concave end arc at +X
end_tool = box(55, 130, -20, 60, -30, 30).intersect(zcyl(END_CX, END_CY, END_R, -30, 30))
body = body.cut(end_tool)

# rounded top/bottom rim of the end face: a ring tool revolved about the arc axis
f = END_FILLET
ring = (cq.Workplane("XZ", origin=(END_CX, END_CY, 0))
        .moveTo(END_R - 1.0, H - f).lineTo(END_R + f, H - f).lineTo(END_R + f, H + 1.0)
        .lineTo(END_R - 1.0, H + 1.0).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
ring = ring.cut(cq.Workplane("XZ", origin=(END_CX, END_CY, 0))
                .moveTo(END_R + f, H - f).circle(f)
                .revolve(360, (0, 0, 0), (0, 1, 0)))
body = body.cut(ring).cut(ring.mirror("XY"))


# lobes at the -X end: for X < X_WALL0 keep only the lobe outline; the lobe is a
# skin of constant thickness under the domed top, thickening through a cone
# (chamfer) towards the eyelet
lobe_cyl = zcyl(LOBE_C[0], LOBE_C[1], LOBE_R, -H - 1, H + 1)
lobe_body = body.intersect(lobe_cyl.intersect(box(-2, X_WALL0 + 1, -20, 60, -30, 30)))
keep = None
for s in (1, -1):
    skin = lobe_body.cut(lobe_body.translate((0, 0, -s * LOBE_SKIN)))
    cone = cq.Workplane("XY").add(cq.Solid.makeCone(
        LOBE_CH_R, LOBE_CH_R + (H + 1 - LIP_IN) * LOBE_CH_SLOPE, H + 1 - LIP_IN,
        pnt=cq.Vector(LOBE_C[0], LOBE_C[1], LIP_IN), dir=cq.Vector(0, 0, 1)))
    if s < 0:
        cone = cone.mirror("XY")
    k = skin.union(cone.intersect(lobe_cyl))
    keep = k if keep is None else keep.union(k)
front_cut = box(-2, X_WALL0, -20, 60, -30, 30).cut(keep)
body = body.cut(front_cut)

# rounded top rim of the lobes (torus ring about the lobe axis, only where the lobe protrudes)
g = LOBE_RND
lring = (cq.Workplane("XZ", origin=(LOBE_C[0], LOBE_C[1], 0))
         .moveTo(LOBE_R - g, H - g).lineTo(LOBE_R + 1.0, H - g).lineTo(LOBE_R + 1.0, H + 1.0)
         .lineTo(LOBE_R - g, H + 1.0).close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
lring = lring.cut(cq.Workplane("XZ", origin=(LOBE_C[0], LOBE_C[1], 0))
                  .moveTo(LOBE_R - g, H - g).circle(g)
                  .revolve(360, (0, 0, 0), (0, 1, 0)))
lring = lring.intersect(box(-2, X_WALL0, -20, 60, -30, 30))
body = body.cut(lring).cut(lring.mirror("XY"))

# open pocket at the -X end (open towards -X and -Y)
pocket = section_prism(-2.0, POCKET_X1, W_SECT[0][1] - WALL_T, (H - WALL_T) / H)
pocket = pocket.intersect(box(-2, POCKET_X1, -20, 60, -LIP_IN, LIP_IN))
pocket = pocket.union(box(-2, POCKET_X1, -20, 16, -LIP_IN, LIP_IN))
# the lips end at LIP_EDGE_Y on the -Y side, with a rounded lower edge
pocket = pocket.union(box(-2, POCKET_X1, -20, LIP_EDGE_Y, -H - 1, H + 1))
body = body.cut(pocket)
rn = LIP_NOSE_R
nose = box(-2, POCKET_X1, LIP_EDGE_Y - 1.0, LIP_EDGE_Y + rn, LIP_IN - 0.5, LIP_IN + rn).cut(
    cq.Workplane("YZ").workplane(offset=-3.0).center(LIP_EDGE_Y + rn, LIP_IN + rn)
    .circle(rn).extrude(POCKET_X1 + 5.0))
body = body.cut(nose).cut(nose.mirror("XY"))


# round both ends of the ribbed panel: vertical rounding that is tangent to the
# panel face and runs out at the hood seam (so nothing overhangs there)
def end_round_tool(x_seam, sgn):
    dy = SEAM[0] - PANEL_Y
    # circle tangent to the panel plane at x_t and passing through (x_seam, SEAM_Y)
    x_t = x_seam + sgn * PANEL_END
    rr = (PANEL_END ** 2 + dy ** 2) / (2.0 * dy)
    cyy = PANEL_Y + rr - 0.05          # dip slightly below the face (avoid tangency)
    x0, x1 = sorted((x_t, x_seam - sgn * 6.0))
    if sgn > 0:
        x0 = x_seam - 0.01
    blk = box(x0, x1, PANEL_Y - 5.0, cyy, -SEAM[1] - 0.01, SEAM[1] + 0.01)
    return blk.cut(zcyl(x_t, cyy, rr, -H - 2, H + 2))


body = body.cut(end_round_tool(POCKET_X1, 1)).cut(end_round_tool(PANEL_X1, -1))

# eyelets on the lip inner faces: ring boss with a blind hole
ring_boss = zcyl(LOBE_C[0], LOBE_C[1], EYE_RING[0], LIP_IN - EYE_RING[1], LIP_IN + 0.5)
body = body.union(ring_boss).union(ring_boss.mirror("XY"))
eye = zcyl(LOBE_C[0], LOBE_C[1], EYE_D / 2, LIP_IN - EYE_RING[1] - 0.5, LIP_IN + 1.5)
body = body.cut(eye).cut(eye.mirror("XY"))

# ------------------------------------------------------------------ ribs
ribs = []
for i in range(RIB_N):
    x = RIB_X0 + i * RIB_PITCH
    wires = []
    for z, w, h, inset in ((-RIB_HALF, 0.3, 0.3, 0.5),
                           (-RIB_HALF * 0.5, RIB_W * 0.85, RIB_H * 0.85, 0.1),
                           (0.0, RIB_W, RIB_H, 0.1),
                           (RIB_HALF * 0.5, RIB_W * 0.85, RIB_H * 0.85, 0.1),
                           (RIB_HALF, 0.3, 0.3, 0.5)):
        c = cq.Vector(x, PANEL_Y + inset, z)
        wires.append(cq.Wire.makeEllipse(w, h, c, cq.Vector(0, 0, 1), cq.Vector(1, 0, 0)))
    ribs.append(cq.Solid.makeLoft(wires, False))
body = body.union(cq.Workplane("XY").add(cq.Compound.makeCompound(ribs)))


# ------------------------------------------------------------------ lugs
def lug_solid(z0, z1):
    x0, x1, y0, y1 = LUG_HEAD
    head = cq.Workplane("XY").workplane(offset=z0).center((x0 + x1) / 2, (y0 + y1) / 2) \
        .sketch().rect(x1 - x0, y1 - y0).vertices().fillet(LUG_HEAD_R).finalize() \
        .extrude(z1 - z0)
    nx0, nx1, ny0, ny1 = LUG_NECK
    lug = head.union(box(nx0, nx1, ny0, ny1, z0, z1))
    # blend the neck into the head on the -Y side
    cx = x0 + LUG_HEAD_R
    cy = y0 + LUG_HEAD_R
    xj = cx - math.sqrt(LUG_HEAD_R ** 2 - (ny0 - cy) ** 2)
    try:
        lug = lug.edges(cq.selectors.BoxSelector((xj - 1, ny0 - 1, z0 - 1), (xj + 1, ny0 + 1, z1 + 1))) \
            .fillet(LUG_BLEND)
    except Exception:
        pass
    return lug


for s in (1, -1):
    if s > 0:
        lug = lug_solid(LUG_Z0, LUG_Z1)
        boss = zcyl(LUG_HOLE[0], LUG_HOLE[1], BOSS_D / 2, LUG_Z0 - BOSS_H, LUG_Z0 + 0.5)
    else:
        lug = lug_solid(-LUG_Z1, -LUG_Z0)
        boss = zcyl(LUG_HOLE[0], LUG_HOLE[1], BOSS_D / 2, -LUG_Z0 - 0.5, -LUG_Z0 + BOSS_H)
    body = body.union(lug).union(boss)

# hinge post between the lugs, with a web back to the end face
post = zcyl(POST_C[0], POST_C[1], POST_R, -LUG_Z0 - 0.5, LUG_Z0 + 0.5).union(
    box(64.0, POST_C[0], POST_C[1] - POST_R, POST_C[1] + POST_R, -LUG_Z0 - 0.5, LUG_Z0 + 0.5))
body = body.union(post)

# cross-shaped passage along X through the housing and the post
for (ya, yb, zh) in SLOTS:
    body = body.cut(box(POCKET_X1 - 1.0, 90.0, ya, yb, -zh, zh))

# lug holes and the clearance notch
body = body.cut(zcyl(LUG_HOLE[0], LUG_HOLE[1], LUG_HOLE_D / 2, -20, 20))
body = body.cut(zcyl(NOTCH_C[0], NOTCH_C[1], NOTCH_R, -20, 20))

# dimple in the bottom face
body = body.cut(zcyl(DIMPLE[0], DIMPLE[1], DIMPLE_D / 2, -H - 2, -H + DIMPLE_DEPTH))

result = body
